import cadquery as cq

# ---------------------------------------------------------------------------
# Enclosure kit laid out flat: open box, its lid / base plate (features up),
# a square mounting bar floating in front of the box and a small disc.
# ---------------------------------------------------------------------------

# ---------------- box ----------------
BOX_W = 100.0        # X
BOX_D = 120.0        # Y
BOX_H = 41.2         # Z
BOX_R = 4.0          # outer vertical corner radius
WALL = 3.0
FLOOR = 3.0
IN_R = 4.5           # inner vertical corner radius
IN_FLOOR_FILLET = 4.0
BOT_FILLET = 1.5
RIM_IN_CH = 2.0      # chamfer on the inner top edge of the wall
RIM_OUT_CH = 0.5     # chamfer on the outer top edge of the wall

FRONT_HOLE_D = 15.2
FRONT_HOLE_X = 0.5
FRONT_HOLE_Z = 21.85

WIN_X0, WIN_X1 = -14.0, 16.0      # window through the back wall
WIN_Z0, WIN_Z1 = 14.5, 28.8
FRAME_X0, FRAME_X1 = -21.5, 21.5  # frame on the inner face of the back wall
FRAME_Z0, FRAME_Z1 = 9.0, 35.6
FRAME_T = 5.0
FRAME_HOLE_D = 1.8
FRAME_HOLES = [(-18.0, 13.2), (-18.0, 30.5), (18.0, 13.2), (18.0, 30.5)]

RING_R = 15.5        # round seat in the floor centre
RING_DEPTH = 1.5
RING_IN_R = 8.25
RING_HOLE_R = 4.2
RING_HOLE_D = 1.5

IBLK_X0 = -38.0      # block on the floor (trimmed by the round seat)
IBLK_W = 13.0
IBLK_Y = -0.8
IBLK_TOP = 9.1
IBLK_HOLES_X = [-33.0, -19.0]
IBLK_HOLE_D = 3.5

FLOOR_HOLE = (36.0, 46.0)   # through hole in the floor (back-right)
FLOOR_HOLE_D = 8.0

LABEL = "scheibrot.sd"  # engraved label on the floor (front-right)
LABEL_C = (27.0, -49.0)
LABEL_SIZE = 3.5
LABEL_DEPTH = 0.4

# ---------------- bar ----------------
BAR_X0, BAR_X1 = -5.0, 72.0
BAR_Y0, BAR_Y1 = -90.0, -77.5
BAR_Z0, BAR_Z1 = 22.4, 34.8
BAR_HOLES_BIG = [-33.5, -19.5]     # offsets from the bar centre
BAR_HOLES_SMALL = [19.5, 33.5]
BAR_HOLE_D_BIG = 4.2
BAR_HOLE_D_SMALL = 3.2

# ---------------- disc ----------------
DISC_C = (70.5, -48.0)
DISC_D = 23.7
DISC_T = 2.0
DISC_HOLE_R = 4.3
DISC_HOLE_D = 2.0

# ---------------- plate (lid) ----------------
PL_C = (138.15, -2.65)   # plate centre (global XY)
PL_W = 95.7
PL_D = 115.7
PL_T = 2.8
PL_R = 4.5
FX, FY = 0.1, -0.45     # offset of the feature layout from the plate centre

SO_D = 6.0
SO_H = 5.2
SO_HOLE_D = 1.8
SO_FLARE_D0 = 7.2        # flared standoffs: base / top diameter
SO_FLARE_D1 = 5.8
STANDOFFS = [(0.1, 33.2), (38.8, 33.2), (-38.3, -15.0), (13.9, -15.0),
             (-38.3, -47.5), (13.9, -47.5)]
FLARED = [(40.1, -15.0), (22.7, -39.4), (40.1, -39.4)]

TAB_X = -0.1
TAB_W = 19.4
TAB_EDGE_GAP = 1.0       # tab front face from the plate front edge
TAB_T = 3.6
TAB_H = 26.6
TAB_HOLE_Z = 18.2
TAB_HOLE_D = 11.4

BLK_X0, BLK_X1 = -41.6, -11.6
BLK_UX0, BLK_UX1 = -38.6, -13.4
BLK_Y = 14.0
BLK_YC = 0.35
BLK_H1 = 12.6
BLK_H2 = 19.7
BLK_HOLES_X = [-33.1, -18.8]
BLK_HOLE_D = 5.0
BLK_CBORE_D = 8.5      # counterbore from the underside
BLK_CBORE_H = 4.0

GATE_X0, GATE_X1 = -46.15, -27.85   # plate-local
GATE_Y0, GATE_Y1 = 31.25, 55.95
GATE_H = 24.2
GATE_LIP_W = 3.5
GATE_LIP_H = 26.6
GATE_TUN_W = 13.8
GATE_TUN_H = 19.1
GATE_R = 2.0
GATE_COVE_R = 1.5
GATE_LIP_HOLES_Y = [38.25, 52.15]


def make_box():
    outer = (cq.Workplane("XY").rect(BOX_W, BOX_D).extrude(BOX_H)
             .edges("|Z").fillet(BOX_R)
             .faces("<Z").edges().fillet(BOT_FILLET)
             .faces(">Z").edges().chamfer(RIM_OUT_CH))
    cavity = (cq.Workplane("XY").workplane(offset=FLOOR)
              .rect(BOX_W - 2 * WALL, BOX_D - 2 * WALL).extrude(BOX_H)
              .edges("|Z").fillet(IN_R)
              .faces("<Z").edges().fillet(IN_FLOOR_FILLET))
    box = outer.cut(cavity)
    # rim: wide chamfer on the inner top edge (outer one done above)
    hx, hy = BOX_W / 2 - WALL + 0.2, BOX_D / 2 - WALL + 0.2
    box = (box.faces(">Z").edges(cq.selectors.BoxSelector(
        (-hx, -hy, BOX_H - 0.1), (hx, hy, BOX_H + 0.1))).chamfer(RIM_IN_CH))

    # window frame on the inner face of the back wall, window through both
    yin = BOX_D / 2 - WALL
    frame = (cq.Workplane("XY")
             .box(FRAME_X1 - FRAME_X0, FRAME_T + 1.0, FRAME_Z1 - FRAME_Z0,
                  centered=(False, False, False))
             .translate((FRAME_X0, yin - FRAME_T, FRAME_Z0)))
    box = box.union(frame)
    win = (cq.Workplane("XY")
           .box(WIN_X1 - WIN_X0, 30, WIN_Z1 - WIN_Z0, centered=(False, True, False))
           .translate((WIN_X0, yin, WIN_Z0)))
    box = box.cut(win)
    fh = (cq.Workplane("XZ", origin=(0, yin - FRAME_T, 0))
          .pushPoints(FRAME_HOLES).circle(FRAME_HOLE_D / 2).extrude(-4.0))
    box = box.cut(fh)

    # round hole in the front wall
    hole = (cq.Workplane("XZ", origin=(0, -BOX_D / 2 - 1, 0))
            .center(FRONT_HOLE_X, FRONT_HOLE_Z).circle(FRONT_HOLE_D / 2)
            .extrude(-(WALL + 2)))
    box = box.cut(hole)

    # block on the floor
    blk = (cq.Workplane("XY").workplane(offset=FLOOR - 0.5)
           .center(IBLK_X0 + 15.0, IBLK_Y).rect(30.0, IBLK_W)
           .extrude(IBLK_TOP - FLOOR + 0.5))
    box = box.union(blk)
    # round seat in the floor centre (also trims the end of the block)
    seat = (cq.Workplane("XY").workplane(offset=FLOOR - RING_DEPTH)
            .circle(RING_R).extrude(20))
    box = box.cut(seat)
    boss = (cq.Workplane("XY").workplane(offset=FLOOR - RING_DEPTH - 0.1)
            .circle(RING_IN_R).extrude(RING_DEPTH - 0.4))
    box = box.union(boss)
    rh = (cq.Workplane("XY").workplane(offset=FLOOR - RING_DEPTH - 0.8)
          .polarArray(RING_HOLE_R, 0, 360, 4).circle(RING_HOLE_D / 2).extrude(3.0))
    box = box.cut(rh)
    bh = (cq.Workplane("XY").workplane(offset=FLOOR)
          .pushPoints([(x, IBLK_Y) for x in IBLK_HOLES_X])
          .circle(IBLK_HOLE_D / 2).extrude(20))
    box = box.cut(bh)

    # through hole in the floor (back-right)
    flh = (cq.Workplane("XY").workplane(offset=-1)
           .center(*FLOOR_HOLE).circle(FLOOR_HOLE_D / 2).extrude(FLOOR + 2))
    box = box.cut(flh)

    # engraved label (skipped silently if no font is available)
    try:
        txt = (cq.Workplane("XY").workplane(offset=FLOOR)
               .center(*LABEL_C)
               .text(LABEL, LABEL_SIZE, -LABEL_DEPTH, kind="bold"))
        if txt.val().isValid():
            box = box.cut(txt)
    except Exception:
        pass
    return box


def make_bar():
    cx = (BAR_X0 + BAR_X1) / 2
    cy = (BAR_Y0 + BAR_Y1) / 2
    bar = (cq.Workplane("XY")
           .box(BAR_X1 - BAR_X0, BAR_Y1 - BAR_Y0, BAR_Z1 - BAR_Z0,
                centered=(False, False, False))
           .translate((BAR_X0, BAR_Y0, BAR_Z0)))
    for offs, d in ((BAR_HOLES_BIG, BAR_HOLE_D_BIG), (BAR_HOLES_SMALL, BAR_HOLE_D_SMALL)):
        holes = (cq.Workplane("XY").workplane(offset=BAR_Z0 - 1)
                 .pushPoints([(cx + dx, cy) for dx in offs]).circle(d / 2)
                 .extrude(BAR_Z1 - BAR_Z0 + 2))
        bar = bar.cut(holes)
    return bar


def make_disc():
    d = cq.Workplane("XY").center(*DISC_C).circle(DISC_D / 2).extrude(DISC_T)
    h = (cq.Workplane("XY").workplane(offset=-1).center(*DISC_C)
         .polarArray(DISC_HOLE_R, 90, 360, 4).circle(DISC_HOLE_D / 2)
         .extrude(DISC_T + 2))
    return d.cut(h)


def f(p):
    """feature layout point -> plate-local point"""
    return (p[0] + FX, p[1] + FY)


def make_plate():
    top = PL_T
    plate = (cq.Workplane("XY").rect(PL_W, PL_D).extrude(PL_T)
             .edges("|Z").fillet(PL_R))

    # plain standoffs
    so = (cq.Workplane("XY").workplane(offset=top - 0.2)
          .pushPoints([f(p) for p in STANDOFFS]).circle(SO_D / 2).extrude(SO_H + 0.2))
    plate = plate.union(so)
    # flared standoffs
    for p in FLARED:
        fl = (cq.Workplane("XY").workplane(offset=top - 0.2).center(*f(p))
              .circle(SO_FLARE_D0 / 2).workplane(offset=SO_H + 0.2)
              .circle(SO_FLARE_D1 / 2).loft())
        plate = plate.union(fl)
    sh = (cq.Workplane("XY").workplane(offset=top + 1.0)
          .pushPoints([f(p) for p in STANDOFFS + FLARED]).circle(SO_HOLE_D / 2)
          .extrude(SO_H))
    plate = plate.cut(sh)

    # upright tab with a large hole, at the front edge
    ty0 = -PL_D / 2 + TAB_EDGE_GAP
    tab = (cq.Workplane("XY")
           .box(TAB_W, TAB_T, TAB_H + 0.2, centered=(True, False, False))
           .translate((TAB_X + FX, ty0, top - 0.2)))
    tab = tab.edges("|Y and >Z").fillet(1.0)
    plate = plate.union(tab)
    th = (cq.Workplane("XZ", origin=(0, ty0 - 1, 0))
          .center(TAB_X + FX, top + TAB_HOLE_Z).circle(TAB_HOLE_D / 2)
          .extrude(-(TAB_T + 2)))
    plate = plate.cut(th)

    # stepped block with two through holes
    blo = (cq.Workplane("XY")
           .box(BLK_X1 - BLK_X0, BLK_Y, BLK_H1 + 0.2, centered=(False, True, False))
           .translate((BLK_X0 + FX, FY + BLK_YC, top - 0.2)))
    bup = (cq.Workplane("XY")
           .box(BLK_UX1 - BLK_UX0, BLK_Y, BLK_H2 - BLK_H1 + 0.2,
                centered=(False, True, False))
           .translate((BLK_UX0 + FX, FY + BLK_YC, top + BLK_H1 - 0.2)))
    plate = plate.union(blo).union(bup)
    bh = (cq.Workplane("XY").workplane(offset=-1)
          .pushPoints([f((x, BLK_YC)) for x in BLK_HOLES_X]).circle(BLK_HOLE_D / 2)
          .extrude(top + BLK_H2 + 2))
    plate = plate.cut(bh)
    cb = (cq.Workplane("XY").workplane(offset=-1)
          .pushPoints([f((x, BLK_YC)) for x in BLK_HOLES_X]).circle(BLK_CBORE_D / 2)
          .extrude(BLK_CBORE_H + 1))
    plate = plate.cut(cb)

    # gate: arch with a tunnel along X and a raised lip along its -X edge
    gw = GATE_X1 - GATE_X0
    gd = GATE_Y1 - GATE_Y0
    gate = (cq.Workplane("XY")
            .box(gw, gd, GATE_H + 0.2, centered=(False, False, False))
            .translate((GATE_X0, GATE_Y0, top - 0.2))
            .edges("|Z").fillet(GATE_R))
    lip = (cq.Workplane("XY")
           .box(GATE_LIP_W, gd, GATE_LIP_H - GATE_H + 0.5, centered=(False, False, False))
           .translate((GATE_X0, GATE_Y0, top + GATE_H - 0.5))
           .edges("|Z and <X").fillet(GATE_R - 0.1))
    gate = gate.union(lip)
    cx = GATE_X0 + GATE_LIP_W
    cz = top + GATE_H
    gate = gate.edges(cq.selectors.BoxSelector(
        (cx - 0.1, GATE_Y0 - 1, cz - 0.1), (cx + 0.1, GATE_Y1 + 1, cz + 0.1))).fillet(GATE_COVE_R)
    ymid = (GATE_Y0 + GATE_Y1) / 2
    tun = (cq.Workplane("XY")
           .box(gw + 10, GATE_TUN_W, GATE_TUN_H + 1, centered=(False, True, False))
           .translate((GATE_X0 - 5, ymid, top - 1)))
    gate = gate.cut(tun)
    lh = (cq.Workplane("XY").workplane(offset=top + GATE_LIP_H - 3)
          .pushPoints([(GATE_X0 + GATE_LIP_W / 2, y) for y in GATE_LIP_HOLES_Y])
          .circle(0.7).extrude(5))
    gate = gate.cut(lh)
    plate = plate.union(gate)

    return plate.translate((PL_C[0], PL_C[1], 0))


box = make_box()
bar = make_bar()
disc = make_disc()
plate = make_plate()

result = (cq.Workplane("XY")
          .newObject([cq.Compound.makeCompound(
              [box.val(), bar.val(), disc.val(), plate.val()])]))

VIEW = {"azimuth": 45, "elevation": 26}
